import cadquery as cq

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- driving dimensions (mm) ----------------
D_BODY = 48.4          # main body outer diameter
L_BODY = 61.7          # main body length (along X, from x = 0)
BODY_BORE_D = 43.15    # main body internal bore

NECK_LEN = 10.7        # length of the male-threaded spigot
NECK_ROOT_D = 40.75    # spigot root diameter
NECK_BORE_D = 37.7     # spigot bore (smallest through bore)
STEP_X = L_BODY - 0.3  # where the spigot bore opens into the body bore
STEP_SLOPE = 1.0       # axial/radial ratio of the conical transition (45 deg)

# male thread on the spigot (right hand helix about +X)
PITCH = 2.9
THREAD_MAJOR_D = 42.55 # crest diameter
CREST_W = 1.3          # crest flat width
TOOTH_BASE_W = 1.7     # tooth width at the root
M_START_X = L_BODY + 2.85   # crest centre at the start of the helix
M_START_ANG = 0.0           # start angle (deg, about +X, 0 = +Y, 90 = +Z)
M_TURN_DEG = 855.0          # swept angle of the male thread

# female thread at the -X end (helical ridge standing in from the bore)
FEM_MINOR_D = 40.95    # ridge crest diameter
FEM_CREST_W = 1.3      # ridge crest width
FEM_BASE_W = 1.7       # ridge width at the bore
F_PITCH = 3.5          # female thread pitch
F_START_X = 2.0        # ridge centre at the start of the helix
F_LEFTHAND = False     # right hand, like the spigot thread
F_START_ANG = 224.0
F_TURN_DEG = 966.0

# cross hole (through both walls, along Z)
HOLE_D = 10.9
HOLE_X = 0.587 * L_BODY

R = D_BODY / 2.0
OUTER_SEAM_ANG = -50.0   # angular position of the revolve seams (deg about +X)
BORE_SEAM_ANG = 128.0
HOLE_SEAM_ANG = 45.0     # seam of the cross hole, turned onto its silhouette


def helical_ring(r_in, r_out, w_in, w_out, x0, ang0, sweep_deg, pitch, lefthand=False):
    """Trapezoid-section helical solid about the +X axis.

    r_in/w_in: radius and axial width of the inner side, r_out/w_out of the outer
    side; x0 is the axial centre at the start angle ang0 (deg)."""
    height = pitch * sweep_deg / 360.0
    r_path = 0.5 * (r_in + r_out)
    path = cq.Wire.makeHelix(pitch, height, r_path, lefthand=lefthand)
    prof = cq.Wire.makePolygon(
        [
            cq.Vector(r_in, 0, -w_in / 2),
            cq.Vector(r_out, 0, -w_out / 2),
            cq.Vector(r_out, 0, w_out / 2),
            cq.Vector(r_in, 0, w_in / 2),
        ],
        close=True,
    )
    solid = cq.Solid.sweep(prof, [], path, makeSolid=True, isFrenet=True)
    # local frame (helix along +Z, starting on +X) -> global (axis +X, start on +Y)
    solid = solid.rotate(cq.Vector(0, 0, 0), cq.Vector(1, 1, 1), 120.0)
    solid = solid.rotate(cq.Vector(0, 0, 0), cq.Vector(1, 0, 0), ang0)
    return solid.translate(cq.Vector(x0, 0, 0))


# ---------------- turned outer form ----------------
# half profiles in the XY plane (Y = radius), revolved about the X axis; the
# revolve seams are turned to where they sit least in view
outer_pts = [
    (0.0, 0.0),
    (0.0, R),
    (L_BODY, R),
    (L_BODY, NECK_ROOT_D / 2),
    (L_BODY + NECK_LEN, NECK_ROOT_D / 2),
    (L_BODY + NECK_LEN, 0.0),
]
outer = (
    cq.Workplane("XY")
    .polyline(outer_pts)
    .close()
    .revolve(360.0, (0, 0, 0), (1, 0, 0))
    .rotate((0, 0, 0), (1, 0, 0), OUTER_SEAM_ANG)
)

# ---------------- stepped through bore ----------------
bore_pts = [
    (-1.0, 0.0),
    (-1.0, BODY_BORE_D / 2),
    (STEP_X - (BODY_BORE_D - NECK_BORE_D) / 2 * STEP_SLOPE, BODY_BORE_D / 2),
    (STEP_X, NECK_BORE_D / 2),
    (L_BODY + NECK_LEN + 1.0, NECK_BORE_D / 2),
    (L_BODY + NECK_LEN + 1.0, 0.0),
]
bore = (
    cq.Workplane("XY")
    .polyline(bore_pts)
    .close()
    .revolve(360.0, (0, 0, 0), (1, 0, 0))
    .rotate((0, 0, 0), (1, 0, 0), BORE_SEAM_ANG)
)
body = outer.cut(bore)

# ---------------- male thread (helical tooth) ----------------
male = helical_ring(
    NECK_ROOT_D / 2 - 0.3, THREAD_MAJOR_D / 2,
    TOOTH_BASE_W + 0.2, CREST_W,
    M_START_X, M_START_ANG, M_TURN_DEG, PITCH,
)
body = body.union(cq.Workplane("XY").add(male))

# ---------------- female thread (helical ridge) ----------------
female = helical_ring(
    FEM_MINOR_D / 2, BODY_BORE_D / 2 + 0.3,
    FEM_CREST_W, FEM_BASE_W + 0.2,
    F_START_X, F_START_ANG, F_TURN_DEG, F_PITCH, lefthand=F_LEFTHAND,
)
body = body.union(cq.Workplane("XY").add(female))

# ---------------- cross hole through both walls ----------------
hole = (
    cq.Workplane("XY", origin=(HOLE_X, 0, -R - 2))
    .circle(HOLE_D / 2)
    .extrude(D_BODY + 4)
    .rotate((HOLE_X, 0, 0), (HOLE_X, 0, 1), HOLE_SEAM_ANG)
)
body = body.cut(hole)

result = body
